import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
R_FLANGE = 50.0        # flange outer radius
R_BODY = 44.0          # body outer radius
H = 46.0               # overall height
Z_RIM = 5.7            # top of the vertical flange rim
Z_JOIN = 12.2          # where the conical flange top meets the body
BOT_CH_H = 0.6         # bottom outer chamfer, radial leg
BOT_CH_V = 1.1         # bottom outer chamfer, vertical leg
TOP_CH_H = 1.8         # top outer chamfer, radial leg
TOP_CH_V = 2.8         # top outer chamfer, vertical leg
TOP_LAND = 0.5         # width of the flat top land of the rim
R_FLOOR = 40.8         # inner radius of the cup at the floor (drafted wall)
Z_FLOOR = 35.1         # height of the recessed floor
R_HOLE = 22.55         # central through-hole radius
Z_HOLE_BOT = 29.3      # virtual corner where hole wall meets the inner cone
R_CONE_BOT = 45.7      # inner cone radius at the bottom
IN_CH = 0.5            # chamfer between inner cone and bottom face
BLEND_R = 3.0          # blend radius between hole wall and inner cone
SEAM_ANGLE = 45.0      # where the revolve seam ends up (deg about Z)

VIEW = {"azimuth": 45, "elevation": 26}

R_TOP_IN = R_BODY - TOP_CH_H - TOP_LAND   # inner radius at the top of the rim

# ---------------- blend between hole wall and underside cone ----------------
corner = (R_HOLE, Z_HOLE_BOT)
cone_end = (R_CONE_BOT, IN_CH)
dx, dz = cone_end[0] - corner[0], cone_end[1] - corner[1]
L = math.hypot(dx, dz)
u2 = (dx / L, dz / L)                      # cone direction (down / outwards)
alpha = math.acos(u2[1])                   # material wedge angle at the corner
t = BLEND_R / math.tan(alpha / 2.0)        # tangent length of the blend arc
T1 = (R_HOLE, Z_HOLE_BOT + t)              # blend start on the hole wall
T2 = (corner[0] + u2[0] * t, corner[1] + u2[1] * t)   # blend end on the cone
bx, bz = u2[0], 1.0 + u2[1]
bl = math.hypot(bx, bz)
dmid = BLEND_R / math.sin(alpha / 2.0) - BLEND_R
MID = (corner[0] + bx / bl * dmid, corner[1] + bz / bl * dmid)

# ---------------- half cross-section (r, z), revolved about Z ----------------
prof = (
    cq.Workplane("XZ")
    .moveTo(R_CONE_BOT + IN_CH, 0.0)
    .lineTo(R_FLANGE - BOT_CH_H, 0.0)          # bottom face of the flange
    .lineTo(R_FLANGE, BOT_CH_V)                # bottom outer chamfer
    .lineTo(R_FLANGE, Z_RIM)                   # flange rim
    .lineTo(R_BODY, Z_JOIN)                    # conical flange top
    .lineTo(R_BODY, H - TOP_CH_V)              # body wall
    .lineTo(R_BODY - TOP_CH_H, H)              # top outer chamfer
    .lineTo(R_TOP_IN, H)                       # top land
    .lineTo(R_FLOOR, Z_FLOOR)                  # drafted inner cup wall
    .lineTo(R_HOLE, Z_FLOOR)                   # recessed floor
    .lineTo(*T1)                               # through-hole wall
    .threePointArc(MID, T2)                    # blend
    .lineTo(R_CONE_BOT, IN_CH)                 # underside cone
    .close()                                   # inner bottom chamfer
)

body = prof.revolve(360.0, (0, 0, 0), (0, 1, 0))

# put the revolve seam where it is least conspicuous
result = body.rotate((0, 0, 0), (0, 0, 1), SEAM_ANGLE)
